import cadquery as cq
import math

# Cartridge shell half (MSX style).  Plate lies in the XZ plane, the open
# (inner) side faces -Y, the outer face with the engraved logo faces +Y.
# Layout positions below are given as (u, v): u measured along +X from the
# left edge, v measured along +Z from the bottom edge.

# ---------------- driving dimensions (mm) ----------------
W = 63.8            # width  (X)
H = 100.0           # height (Z)
T = 7.5             # rim plane -> outer face thickness (Y)
RAISE = 0.6         # raised blocks stand proud of the rim plane
FLOOR_T = 1.9       # main pocket floor thickness
STRIP_FLOOR_T = 1.9 # connector strip floor thickness
LEDGE_D = 2.3       # depth of the rim ledge below the rim plane
RIM_UP = 1.4        # rim thickness above the ledge
RIM_LO = 2.4        # rim thickness below the ledge
R_OUT_LEFT = 2.3    # plan corner radius, left corners
R_FACE = 0.7        # fillet around outer face (not on the connector edge)
HOLE_CSK = 0.5      # chamfer on the outer end of the through hole

WALL_X0 = 53.3      # separating wall left face
WALL_X1 = 54.65     # separating wall right face
WALL_TOP_V0 = 76.2  # raised upper wall section start
WALL_BOT_V1 = 15.0  # raised lower wall section end
STRIP_Z0 = 5.4      # connector opening bottom
STRIP_Z1 = 85.6     # connector opening top
BOT_BLOCK_V0 = 3.6  # raised bottom block lower edge (next to the wall)
BOT_NOTCH_U1 = 61.8 # end of the rim groove running under the bottom block

HOLE_U, HOLE_V = 47.7, 92.15
HOLE_D = 6.1
HOLE_BOSS_R = 4.3
BLOCK_V0 = 87.85
BLOCK_TOP = 98.75
SLOT_U1 = 61.5      # end of the shallow notch between block and top rim
SLOT_DEPTH = 1.1    # notch depth below the raised block face
SLOT_GAP = 0.85     # notch starts this far above the hole boss
CH_R = 2.8
CH_U0 = 52.6

BOSSES = [(43.3, 71.4), (48.1, 19.9)]
BOSS_D = 5.5
LUG_W = 1.9
LUG_R = 3.9
LUG_DROP = 0.7      # lugs stop short of the boss end face
PIN_D = 3.9
PIN_L = 1.7
LUG_FILLET = 0.5
PIN_HOLE_D = 1.7

RECT = (5.2, 25.3, 6.4, 93.7)   # shallow label recess on inner floor
RECT_DEPTH = 0.7
RECT_R = 0.3

SIDE_RECESS = 0.65              # -X side face relief
SIDE_RECESS_V = (12.4, 87.5)
SIDE_REBATE_W = 4.4             # rebate along the outer face, left edge
SIDE_REBATE_D = 0.8

# engraving on the outer face (logo frame, insertion arrow, lettering)
ENG_W = 0.5
ENG_D = 0.3
FRAME = (25.8, 50.0, 12.3, 87.0)      # u0, u1, v0, v1
FRAME_RIGHT_SEGS = [(13.9, 25.5), (73.8, 85.4)]
ARROW = ((54.1, 30.1), (54.1, 72.5), (60.3, 51.3))
LOGO_TEXT = "MSX"
LOGO_CENTER = (37.5, 57.8)            # (u, v) of the lettering centre
LOGO_SIZE = 20.0
SUB_TEXT = "eq"
SUB_CENTER = (42.0, 22.5)
SUB_SIZE = 12.5

# snap windows in the rim upper wall
SNAP_DEPTH = 0.6
SNAP_D0 = 0.9
LEFT_SNAPS = [(20.1, 34.2), (65.5, 79.4)]
TOPBOT_SNAP = (24.0, 38.5)

# Y levels
y_out = T / 2.0
y_rim = -T / 2.0
y_raise = y_rim - RAISE
y_floor = y_out - FLOOR_T
y_sfloor = y_out - STRIP_FLOOR_T
y_ledge = y_rim + LEDGE_D


def X(u):
    return u - W / 2.0


def Z(v):
    return v - H / 2.0


def box(u0, u1, y0, y1, v0, v1):
    return (cq.Workplane("XY")
            .box(u1 - u0, y1 - y0, v1 - v0, centered=False)
            .translate((X(u0), y0, Z(v0))))


def ycyl(u, v, r, y0, y1):
    """cylinder with axis along Y from y0 to y1"""
    return (cq.Workplane("XZ", origin=(0, y1, 0))
            .center(X(u), Z(v)).circle(r).extrude(y1 - y0))


# ---------------- base body ----------------
body = box(0, W, y_rim, y_out, 0, H)
body = body.edges("|Y").edges("<X").fillet(R_OUT_LEFT)
body = body.faces(">Y").edges("not >X").fillet(R_FACE)

# ---------------- main pocket (two stepped levels) ----------------
up = box(RIM_UP, WALL_X0, y_rim - 1, y_ledge, RIM_UP, H - RIM_UP)
up = up.edges("|Y").edges("<X").fillet(R_OUT_LEFT - RIM_UP + 0.3)
lo = box(RIM_LO, WALL_X0, y_rim - 1, y_floor, RIM_LO, H - RIM_LO)
lo = lo.edges("|Y").fillet(0.6)
body = body.cut(up).cut(lo)

# connector strip opening (open to +X and to the inner side)
strip = box(WALL_X1, W + 1, y_rim - 1, y_sfloor, STRIP_Z0, STRIP_Z1)
body = body.cut(strip)

# ---------------- hole / channel block ----------------
blk = (cq.Workplane("XZ", origin=(0, y_floor, 0))
       .center(X(HOLE_U), Z(HOLE_V)).circle(HOLE_BOSS_R)
       .extrude(y_floor - y_raise))
blk = blk.union(box(HOLE_U, W, y_raise, y_floor, BLOCK_V0, HOLE_V + HOLE_BOSS_R))
blk = blk.union(box(WALL_X0, W, y_raise, y_floor, STRIP_Z1, BLOCK_TOP))
blk = blk.cut(box(WALL_X0 - 1, SLOT_U1, y_raise - 1, y_raise + SLOT_DEPTH,
                  HOLE_V + HOLE_BOSS_R + SLOT_GAP, H))
body = body.union(blk)

# raised wall sections top and bottom
body = body.union(box(WALL_X0, WALL_X1, y_raise, y_floor, WALL_TOP_V0, BLOCK_V0 + 0.1))
body = body.union(box(WALL_X0, WALL_X1, y_raise, y_floor, BOT_BLOCK_V0, WALL_BOT_V1))
# raised bottom block (stands proud of the rim)
body = body.union(box(WALL_X0, W, y_raise, y_rim + 0.01, BOT_BLOCK_V0, STRIP_Z0))
body = body.union(box(BOT_NOTCH_U1, W, y_raise, y_rim + 0.01, RIM_UP, STRIP_Z0))
# groove continuing the bottom rim step under the bottom block
body = body.cut(box(WALL_X0, BOT_NOTCH_U1, y_raise - 1, y_ledge, RIM_UP, BOT_BLOCK_V0))

# through hole
body = body.cut(ycyl(HOLE_U, HOLE_V, HOLE_D / 2, y_raise - 1, y_out + 1))
csk = cq.Solid.makeCone(HOLE_D / 2 + HOLE_CSK + 1.0, HOLE_D / 2 - 0.01, HOLE_CSK + 1.01,
                        pnt=cq.Vector(X(HOLE_U), y_out + 1.0, Z(HOLE_V)),
                        dir=cq.Vector(0, -1, 0))
body = body.cut(cq.Workplane("XY").add(csk))
csk2 = cq.Solid.makeCone(HOLE_D / 2 + HOLE_CSK + 1.0, HOLE_D / 2 - 0.01, HOLE_CSK + 1.01,
                         pnt=cq.Vector(X(HOLE_U), y_raise - 1.0, Z(HOLE_V)),
                         dir=cq.Vector(0, 1, 0))
body = body.cut(cq.Workplane("XY").add(csk2))
# half-round channel
ch = (cq.Workplane("YZ", origin=(X(CH_U0), 0, 0))
      .center(y_raise, Z(HOLE_V)).circle(CH_R).extrude(W - CH_U0 + 1))
body = body.cut(ch)

# ---------------- screw bosses ----------------
for (bu, bv) in BOSSES:
    b = ycyl(bu, bv, BOSS_D / 2, y_rim, y_floor + 0.2)
    for ang in (0, 90, 180, 270):
        lug = (cq.Workplane("XY")
               .box(LUG_R, y_floor + 0.2 - (y_rim + LUG_DROP), LUG_W,
                    centered=(False, False, True))
               .edges("|Y and >X").fillet(LUG_FILLET)
               .translate((0, y_rim + LUG_DROP, 0))
               .rotate((0, 0, 0), (0, 1, 0), -ang)
               .translate((X(bu), 0, Z(bv))))
        b = b.union(lug)
    pin = (cq.Workplane("XZ", origin=(0, y_rim + 0.1, 0))
           .center(X(bu), Z(bv)).circle(PIN_D / 2).extrude(PIN_L + 0.1))
    b = b.union(pin)
    body = body.union(b)
    body = body.cut(ycyl(bu, bv, PIN_HOLE_D / 2, y_rim - PIN_L - 1, y_floor - 0.5))

# ---------------- shallow label recess on the inner floor ----------------
r = box(RECT[0], RECT[1], y_floor - 0.01, y_floor + RECT_DEPTH, RECT[2], RECT[3])
r = r.edges("|Y").fillet(RECT_R)
body = body.cut(r)

# ---------------- snap windows in the rim upper wall ----------------
for (v0, v1) in LEFT_SNAPS:
    body = body.cut(box(RIM_UP - SNAP_DEPTH, RIM_UP + 0.01,
                        y_rim + SNAP_D0, y_ledge + 0.01, v0, v1))
u0, u1 = TOPBOT_SNAP
body = body.cut(box(u0, u1, y_rim + SNAP_D0, y_ledge + 0.01,
                    RIM_UP - SNAP_DEPTH, RIM_UP + 0.01))
body = body.cut(box(u0, u1, y_rim + SNAP_D0, y_ledge + 0.01,
                    H - RIM_UP - 0.01, H - RIM_UP + SNAP_DEPTH))

# ---------------- side relief on -X face ----------------
body = body.cut(box(-1, SIDE_RECESS, y_raise - 1, y_out + 1,
                    SIDE_RECESS_V[0], SIDE_RECESS_V[1]))

# rebate along the outer face at the left edge (same span as the relief)
body = body.cut(box(-1, SIDE_REBATE_W, y_out - SIDE_REBATE_D, y_out + 1,
                    SIDE_RECESS_V[0], SIDE_RECESS_V[1]))


# ---------------- outer face engraving ----------------
def groove(p0, p1, w=ENG_W, d=ENG_D):
    (u0, v0), (u1, v1) = p0, p1
    L = math.hypot(u1 - u0, v1 - v0)
    ang = math.degrees(math.atan2(v1 - v0, u1 - u0))
    g = (cq.Workplane("XY")
         .box(L + w, d + 1.0, w)
         .rotate((0, 0, 0), (0, 1, 0), -ang)
         .translate((X((u0 + u1) / 2), y_out - d + (d + 1.0) / 2, Z((v0 + v1) / 2))))
    return g


fu0, fu1, fv0, fv1 = FRAME
eng = groove((fu1, fv0), (fu1, fv1))
eng = eng.union(groove((fu0, fv1), (fu1, fv1)))
eng = eng.union(groove((fu0, fv0), (fu1, fv0)))
for (a, b) in FRAME_RIGHT_SEGS:
    eng = eng.union(groove((fu0, a), (fu0, b)))
a0, a1, a2 = ARROW
eng = eng.union(groove(a0, a1)).union(groove(a1, a2)).union(groove(a2, a0))
body = body.cut(eng)

# lettering: reads along -Z with its top towards -X (plain font), engraved as
# shallow pockets in the outer face


def filled_letters(txt_s, cu, cv, size, kind):
    tp = cq.Plane(origin=(X(cu), y_out + 0.5, Z(cv)), xDir=(0, 0, -1), normal=(0, 1, 0))
    return [cq.Workplane(tp).text(txt_s, size, -(ENG_D + 0.5), kind=kind,
                                  combine=False).val()]


for (txt_s, (cu, cv), size, kind) in (
        (LOGO_TEXT, LOGO_CENTER, LOGO_SIZE, "bold"),
        (SUB_TEXT, SUB_CENTER, SUB_SIZE, "regular")):
    try:
        cut_body = body
        for g in filled_letters(txt_s, cu, cv, size, kind):
            cut_body = cut_body.cut(cq.Workplane("XY").add(g))
        if cut_body.val().isValid() and len(cut_body.solids().vals()) == 1:
            body = cut_body
    except Exception:
        pass

result = body
